import math
import cadquery as cq

# ---------------------------------------------------------------------------
# Lattice bridge-pier / signal tower block.
# All driving dimensions are given in "grid units" (U) and scaled to mm.
# X = width, Y = depth (back face of tower at Y=0, front toward -Y), Z = up.
# ---------------------------------------------------------------------------
U = 0.25  # mm per grid unit

W = 117.5          # overall width (X)
HW = W / 2.0
H_TOWER = 200.75   # top of the lattice tower (underside of cap at back)
D_BOT = 85.25      # depth of the footprint (front flare at bottom)
D_TOP = 45.5       # depth of tower at its top
ARC_MID = (-54.5, 100.0)  # point on the concave front flare (y, z)

CAP_Z0 = 212.25    # underside of cap at the front
CAP_Z1 = 237.0     # top of cap
CAP_FRONT = -48.5  # cap front face (y)
CAP_BACK = 22.25   # cap back face (y)
CAP_R_BACK = 17.0  # big round on top-back edge
CAP_R_FRONT = 5.0  # small round on top-front edge
CAP_CHAMF_Z = 210.25  # start of the lower back chamfer
CAP_CHAMF_Y = 9.25
NOTCH_HW = 32.3    # half-width of the notch in the cap back

POCKET = 4.0       # depth of lattice pockets
MEMBER = 6.5       # width of lattice diagonals
COL = 6.25         # corner column width seen on front/back faces
SIDE_FRONT = 7.0   # front chord width on the side faces (horizontal)
SIDE_BACK = 9.0    # back chord width on the side faces

HOLE_D = 18.0      # fixing holes
HOLE_CSK = 22.0
HOLE_DEPTH = 7.0


def s(v):
    return v * U


# ---------------------------------------------------------------------------
# helpers (all coordinates in grid units)
# ---------------------------------------------------------------------------
def prism_xz(pts, y0, y1):
    """Prism with polygon pts=(x,z) in the XZ plane spanning y0..y1."""
    wp = cq.Workplane("XZ", origin=(0, s(y1), 0))
    return wp.polyline([(s(a), s(b)) for a, b in pts]).close().extrude(s(y1 - y0))


def prism_yz(pts, x0, x1):
    """Prism with polygon pts=(y,z) in the YZ plane spanning x0..x1."""
    wp = cq.Workplane("YZ", origin=(s(x0), 0, 0))
    return wp.polyline([(s(a), s(b)) for a, b in pts]).close().extrude(s(x1 - x0))


def bar_pts(p1, p2, w, ext=6.0):
    (x1, z1), (x2, z2) = p1, p2
    dx, dz = x2 - x1, z2 - z1
    L = math.hypot(dx, dz)
    ux, uz = dx / L, dz / L
    nx, nz = -uz * w / 2.0, ux * w / 2.0
    ax, az = x1 - ux * ext, z1 - uz * ext
    bx, bz = x2 + ux * ext, z2 + uz * ext
    return [(ax + nx, az + nz), (bx + nx, bz + nz), (bx - nx, bz - nz), (ax - nx, az - nz)]


POCKET_R = 0.6  # corner round of the lattice pockets


def round_edges(wp, sel, r=POCKET_R):
    try:
        out = wp.edges(sel).fillet(s(r))
        if out.val().isValid():
            return out
    except Exception:
        pass
    return wp


def rect_pts(x0, z0, x1, z1):
    return [(x0, z0), (x1, z0), (x1, z1), (x0, z1)]


# front flare circle through three points (y,z)
def _circle(p1, p2, p3):
    (x1, y1), (x2, y2), (x3, y3) = p1, p2, p3
    a = [[2 * x1, 2 * y1, 1.0], [2 * x2, 2 * y2, 1.0], [2 * x3, 2 * y3, 1.0]]
    b = [x1 * x1 + y1 * y1, x2 * x2 + y2 * y2, x3 * x3 + y3 * y3]
    # cramer
    def det(m):
        return (m[0][0] * (m[1][1] * m[2][2] - m[1][2] * m[2][1])
                - m[0][1] * (m[1][0] * m[2][2] - m[1][2] * m[2][0])
                + m[0][2] * (m[1][0] * m[2][1] - m[1][1] * m[2][0]))
    d = det(a)
    res = []
    for i in range(3):
        m = [row[:] for row in a]
        for r in range(3):
            m[r][i] = b[r]
        res.append(det(m) / d)
    cx, cy, c = res
    return cx, cy, math.sqrt(c + cx * cx + cy * cy)


P_BOT = (-D_BOT, 0.0)
P_TOP = (-D_TOP, H_TOWER)
FC_Y, FC_Z, FC_R = _circle(P_BOT, ARC_MID, P_TOP)


def front_y(z):
    """y of the curved front face at height z."""
    z = min(z, FC_Z)
    return FC_Y + math.sqrt(FC_R ** 2 - (z - FC_Z) ** 2)


# ---------------------------------------------------------------------------
# tower body (side profile extruded across the width)
# ---------------------------------------------------------------------------
Z_TOWER_TOP = 220.0


def tower_profile_solid(dy=0.0):
    wp = cq.Workplane("YZ", origin=(s(-HW), 0, 0))
    prof = (wp.moveTo(s(0 + dy), 0)
            .lineTo(s(-D_BOT + dy), 0)
            .threePointArc((s(ARC_MID[0] + dy), s(ARC_MID[1])), (s(-D_TOP + dy), s(H_TOWER)))
            .lineTo(s(-D_TOP + dy), s(Z_TOWER_TOP))
            .lineTo(s(0 + dy), s(Z_TOWER_TOP))
            .close())
    return prof.extrude(s(W))


body = tower_profile_solid()

# ---------------------------------------------------------------------------
# FRONT lattice (pattern drawn in the XZ projection, cut normal to the flare)
# ---------------------------------------------------------------------------
XI = HW - COL            # inner edge of corner columns
F_TOP = H_TOWER
F_N1 = 133.0             # side node between the two X panels
F_HM = (45.6, 49.8)      # horizontal member above the W truss
F_HB = (19.7, 24.8)      # horizontal member above the base band
F_NODE = 47.7
F_WB = 22.25
F_WX = 20.0
NODE_HX, NODE_HZ = 9.25, 5.8

front_bars = [
    bar_pts((-XI, F_TOP), (XI, F_N1), MEMBER),
    bar_pts((XI, F_TOP), (-XI, F_N1), MEMBER),
    bar_pts((-XI, F_N1), (XI, F_NODE), MEMBER),
    bar_pts((XI, F_N1), (-XI, F_NODE), MEMBER),
    bar_pts((-XI, F_NODE), (-F_WX, F_WB), MEMBER),
    bar_pts((-F_WX, F_WB), (0, F_NODE), MEMBER),
    bar_pts((0, F_NODE), (F_WX, F_WB), MEMBER),
    bar_pts((F_WX, F_WB), (XI, F_NODE), MEMBER),
]
c1 = (F_TOP + F_N1) / 2.0
c2 = (F_N1 + F_NODE) / 2.0
front_nodes = [rect_pts(-NODE_HX, c1 - NODE_HZ, NODE_HX, c1 + NODE_HZ)]  # gusset at upper crossing only

Y_FAR0, Y_FAR1 = -120.0, 40.0
area_x = prism_xz(rect_pts(-XI, F_HM[1], XI, F_TOP), Y_FAR0, Y_FAR1)
for bp in front_bars[:4]:
    area_x = area_x.cut(prism_xz(bp, Y_FAR0 - 1, Y_FAR1 + 1))
for npts in front_nodes:
    area_x = area_x.cut(prism_xz(npts, Y_FAR0 - 1, Y_FAR1 + 1))
area_w = prism_xz(rect_pts(-XI, F_HB[1], XI, F_HM[0]), Y_FAR0, Y_FAR1)
for bp in front_bars[4:]:
    area_w = area_w.cut(prism_xz(bp, Y_FAR0 - 1, Y_FAR1 + 1))
front_area = round_edges(area_x.union(area_w), "|Y")

front_skin = body.cut(tower_profile_solid(POCKET))
body = body.cut(front_area.intersect(front_skin))

# shallow base band at the foot of the front face
BAND_DEPTH = 2.0
band_skin = body.cut(tower_profile_solid(BAND_DEPTH))
band_area = prism_xz(rect_pts(-XI, -1.0, XI, F_HB[0]), Y_FAR0, Y_FAR1)
body = body.cut(band_area.intersect(band_skin))

# ---------------------------------------------------------------------------
# SIDE lattice (both sides; curved front chord)
# ---------------------------------------------------------------------------
S_PANELS = [(171.15, 200.75), (135.25, 166.45), (91.15, 130.0), (48.4, 86.45), (1.5, 43.45)]
S_BACK_IN = -SIDE_BACK
S_STRUT = 4.7  # horizontal strut thickness on the side faces
S_DIAG = 5.6   # diagonal width on the side faces


def side_cutter(x0, x1):
    inner = tower_profile_solid(SIDE_FRONT)  # front chord region removed
    cut = None
    for zb, zt in S_PANELS:
        band = prism_yz(rect_pts(-120.0, zb, S_BACK_IN, zt), x0, x1)
        yf = front_y(zt) + SIDE_FRONT
        # diagonal runs between the chords, its ends on the centre lines of the struts
        zt_n = zt + (S_STRUT / 2.0 if zt < S_PANELS[0][1] else 0.0)
        zb_n = zb - (S_STRUT / 2.0 if zb > S_PANELS[-1][0] else 0.0)
        diag = prism_yz(bar_pts((yf, zt_n), (S_BACK_IN, zb_n), S_DIAG), x0 - 1, x1 + 1)
        piece = band.cut(diag)
        cut = piece if cut is None else cut.union(piece)
    slab = cq.Workplane("XY").box(s(x1 - x0), s(400), s(400), centered=(False, True, False)).translate((s(x0), 0, 0))
    return round_edges(cut.intersect(inner).intersect(slab), "|X")


body = body.cut(side_cutter(HW - POCKET, HW + 1.0))
body = body.cut(side_cutter(-HW - 1.0, -HW + POCKET))

# ---------------------------------------------------------------------------
# BACK lattice
# ---------------------------------------------------------------------------
B_TOP = 180.0
B_N1 = 112.3
B_BOT = 48.2
back_bars = [
    bar_pts((-XI, B_TOP), (XI, B_N1), MEMBER),
    bar_pts((XI, B_TOP), (-XI, B_N1), MEMBER),
    bar_pts((-XI, B_N1), (XI, B_BOT), MEMBER),
    bar_pts((XI, B_N1), (-XI, B_BOT), MEMBER),
]
back_area = prism_xz(rect_pts(-XI, B_BOT, XI, B_TOP), -POCKET, 1.0)
for bp in back_bars:
    back_area = back_area.cut(prism_xz(bp, -POCKET - 1, 2.0))
body = body.cut(round_edges(back_area, "|Y"))

# ---------------------------------------------------------------------------
# CAP
# ---------------------------------------------------------------------------
cap_wp = cq.Workplane("YZ", origin=(s(-HW), 0, 0))
cap = (cap_wp.moveTo(s(CAP_FRONT), s(CAP_Z0))
       .lineTo(s(CAP_FRONT), s(CAP_Z1 - CAP_R_FRONT))
       .radiusArc((s(CAP_FRONT + CAP_R_FRONT), s(CAP_Z1)), s(CAP_R_FRONT))
       .lineTo(s(CAP_BACK - CAP_R_BACK), s(CAP_Z1))
       .radiusArc((s(CAP_BACK), s(CAP_Z1 - CAP_R_BACK)), s(CAP_R_BACK))
       .lineTo(s(CAP_BACK), s(CAP_CHAMF_Z))
       .lineTo(s(CAP_CHAMF_Y), s(H_TOWER))
       .lineTo(s(-D_TOP), s(H_TOWER))
       .lineTo(s(-D_TOP), s(CAP_Z0))
       .close()
       .extrude(s(W)))
notch = cq.Workplane("XY").box(s(2 * NOTCH_HW), s(40), s(60), centered=(True, False, False)).translate((0, 0, s(H_TOWER - 5)))
cap = cap.cut(notch)
body = body.union(cap)

# ---------------------------------------------------------------------------
# CORBELS (front and back)
# ---------------------------------------------------------------------------
F_RIB_N = 12
F_RIB_W = 2.2
F_RIB_OUT = 1.6
f_pitch = (2 * (HW - 5.8)) / (F_RIB_N - 1)
for i in range(F_RIB_N):
    x = -(HW - 5.8) + i * f_pitch
    rib = prism_xz(rect_pts(x - F_RIB_W / 2, H_TOWER, x + F_RIB_W / 2, CAP_Z0), -D_TOP - F_RIB_OUT, -D_TOP + 0.5)
    body = body.union(rib)

B_RIB_Z0 = 181.5      # underside of the back corbels
B_RIB_OUT = 5.3       # projection of the back corbels
B_RIB_TAPER = 3.0     # corbel underside rises this much toward its tip
B_RIB_W = 3.3
B_RIB_PITCH = 10.7
B_LEDGE_OUT = 2.95    # ledge along the foot of the notch wall
B_LEDGE_Z0 = 195.5
B_LEDGE_Z1 = H_TOWER + 0.5  # ledge top flush with the corbel tops
B_END_X0 = 51.85      # wide corbel blocks at the two back corners


def back_corbel(xa, xb):
    prof = [(0.0, B_RIB_Z0), (B_RIB_OUT, B_RIB_Z0 + B_RIB_TAPER),
            (B_RIB_OUT, H_TOWER + 0.5), (-0.5, H_TOWER + 0.5), (-0.5, B_RIB_Z0)]
    return prism_yz(prof, xa, xb)


for i in range(-4, 5):
    x = i * B_RIB_PITCH
    body = body.union(back_corbel(x - B_RIB_W / 2, x + B_RIB_W / 2))
body = body.union(back_corbel(B_END_X0, HW))
body = body.union(back_corbel(-HW, -B_END_X0))
body = body.union(prism_xz(rect_pts(-NOTCH_HW, B_LEDGE_Z0, NOTCH_HW, B_LEDGE_Z1), -0.5, B_LEDGE_OUT))

# ---------------------------------------------------------------------------
# WINDOW GRIDS (3 x 3 small square recesses)
# ---------------------------------------------------------------------------
WIN_SQ = 3.1
WIN_PITCH = 3.8
WIN_DEPTH = 3.0
WIN_Z = 223.0


def window_grid_xz(xc, zc, y0, y1):
    """3x3 grid of square recesses on a face normal to Y, cut between y0..y1."""
    out = None
    for i in (-1, 0, 1):
        for j in (-1, 0, 1):
            x = xc + i * WIN_PITCH
            z = zc + j * WIN_PITCH
            p = prism_xz(rect_pts(x - WIN_SQ / 2, z - WIN_SQ / 2, x + WIN_SQ / 2, z + WIN_SQ / 2), y0, y1)
            out = p if out is None else out.union(p)
    return out


def window_grid_yz(yc, zc, x0, x1):
    """3x3 grid of square recesses on a face normal to X, cut between x0..x1."""
    out = None
    for i in (-1, 0, 1):
        for j in (-1, 0, 1):
            y = yc + i * WIN_PITCH
            z = zc + j * WIN_PITCH
            p = prism_yz(rect_pts(y - WIN_SQ / 2, z - WIN_SQ / 2, y + WIN_SQ / 2, z + WIN_SQ / 2), x0, x1)
            out = p if out is None else out.union(p)
    return out


WIN_FRONT_PITCH = 21.2  # five windows across the cap front
WIN_SIDE_Y = -15.9      # one window on each cap end
WIN_NOTCH_X = 23.6      # one window in the notch wall at the back
for k in range(-2, 3):
    body = body.cut(window_grid_xz(k * WIN_FRONT_PITCH, WIN_Z, CAP_FRONT - 0.5, CAP_FRONT + WIN_DEPTH))
body = body.cut(window_grid_yz(WIN_SIDE_Y, WIN_Z, HW - WIN_DEPTH, HW + 0.5))
body = body.cut(window_grid_yz(WIN_SIDE_Y, WIN_Z, -HW - 0.5, -HW + WIN_DEPTH))
body = body.cut(window_grid_xz(WIN_NOTCH_X, WIN_Z - 2.0, -WIN_DEPTH, 0.5))

# ---------------------------------------------------------------------------
# FIXING HOLES (back face and underside)
# ---------------------------------------------------------------------------
HOLE_X = 29.5
HOLE_BACK_Z = 21.7
HOLE_BOT_Y = -57.0
csk = (HOLE_CSK - HOLE_D) / 2.0
for x in (-HOLE_X, HOLE_X):
    hb = (cq.Workplane("XZ", origin=(s(x), s(1.0), s(HOLE_BACK_Z)))
          .circle(s(HOLE_D / 2)).extrude(s(HOLE_DEPTH + 1.0)))
    body = body.cut(hb)
    cone = cq.Solid.makeCone(s(HOLE_CSK / 2 + 1.0), s(HOLE_D / 2), s(csk + 1.0),
                             pnt=cq.Vector(s(x), s(1.0), s(HOLE_BACK_Z)), dir=cq.Vector(0, -1, 0))
    body = body.cut(cq.Workplane().add(cone))
    hu = (cq.Workplane("XY", origin=(s(x), s(HOLE_BOT_Y), s(-1.0)))
          .circle(s(HOLE_D / 2)).extrude(s(HOLE_DEPTH + 1.0)))
    body = body.cut(hu)
    cone2 = cq.Solid.makeCone(s(HOLE_CSK / 2 + 1.0), s(HOLE_D / 2), s(csk + 1.0),
                              pnt=cq.Vector(s(x), s(HOLE_BOT_Y), s(-1.0)), dir=cq.Vector(0, 0, 1))
    body = body.cut(cq.Workplane().add(cone2))

# ---------------------------------------------------------------------------
# small equipment boxes standing at the foot of the front face
# ---------------------------------------------------------------------------
BOX_FRONT = -77.6   # vertical front face of the two thin plates
BOX_BACK = -74.8    # plates stand free of the receding face
box1 = prism_xz(rect_pts(-3.5, F_HB[0], 18.5, 27.8), BOX_FRONT, BOX_BACK)
box2 = prism_xz([(21.0, F_HB[0]), (51.5, F_HB[0]), (51.5, 32.3), (37.5, 32.3), (36.0, 34.8), (21.0, 34.8)],
                BOX_FRONT, BOX_BACK)
body = body.union(box1).union(box2)

result = body

VIEW = {"azimuth": 45, "elevation": 26}
